import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
W = 120.0          # outer width (square, X and Y)
H = 28.6           # overall height
R_OUT = 7.5        # outer vertical corner radius
T_WALL = 1.6       # wall thickness
T_FLOOR = 2.2      # floor thickness
R_BOT = 0.4        # outer bottom edge fillet
R_TOP = 0.4        # outer top edge fillet
R_FLOOR = 2.0      # inner floor / wall fillet

# screw posts (4, near the corners, free standing)
POST_OFF = 9.0     # post axis offset from outer faces
POST_D = 5.0       # post outer diameter
POST_TOP_DROP = 0.25  # post top below the rim
BASE_D = 9.0       # base disc diameter
BASE_R = 1.9       # concave fillet radius of the base disc (= its height)
POST_R = 0.3       # small fillet between post and base disc
HOLE_D = 2.4       # screw hole diameter
HOLE_CH_D = 3.6    # chamfer outer diameter at the post top
HOLE_DEPTH = 18.0  # screw hole depth
POST_CH = 0.3      # chamfer on the outer top edge of the post

# cable hole in the front wall (-Y)
SIDE_HOLE_D = 15.0
SIDE_HOLE_Z = H / 2.0

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- outer body ----------------
body = (
    cq.Workplane("XY")
    .box(W, W, H, centered=(True, True, False))
    .edges("|Z").fillet(R_OUT)
)
body = body.faces("<Z").edges().fillet(R_BOT)
body = body.faces(">Z").edges().fillet(R_TOP)

# ---------------- inner pocket ----------------
Wi = W - 2 * T_WALL
pocket = (
    cq.Workplane("XY")
    .box(Wi, Wi, H, centered=(True, True, False))
    .edges("|Z").fillet(R_OUT - T_WALL)
)
pocket = pocket.faces("<Z").edges().fillet(R_FLOOR)
pocket = pocket.translate((0, 0, T_FLOOR))
body = body.cut(pocket)

# ---------------- screw posts ----------------
z_f = T_FLOOR
z_top = H - POST_TOP_DROP
rb = BASE_D / 2.0
rp = POST_D / 2.0
k = 1.0 - math.sqrt(0.5)

post_prof = (
    cq.Workplane("XZ")
    .moveTo(0, z_f - 0.8)
    .lineTo(rb + BASE_R, z_f - 0.8)
    .lineTo(rb + BASE_R, z_f)
    .threePointArc((rb + BASE_R * k, z_f + BASE_R * k), (rb, z_f + BASE_R))
    .lineTo(rp + POST_R, z_f + BASE_R)
    .threePointArc((rp + POST_R * k, z_f + BASE_R + POST_R * k), (rp, z_f + BASE_R + POST_R))
    .lineTo(rp, z_top - POST_CH)
    .lineTo(rp - POST_CH, z_top)
    .lineTo(0, z_top)
    .close()
)
post = post_prof.revolve(360, (0, 0, 0), (0, 1, 0))

# hole with a conical countersink at the top
ch = (HOLE_CH_D - HOLE_D) / 2.0
hole_prof = (
    cq.Workplane("XZ")
    .moveTo(0, z_top - HOLE_DEPTH)
    .lineTo(HOLE_D / 2.0, z_top - HOLE_DEPTH)
    .lineTo(HOLE_D / 2.0, z_top - ch)
    .lineTo(HOLE_CH_D / 2.0, z_top)
    .lineTo(HOLE_CH_D / 2.0, z_top + 1.0)
    .lineTo(0, z_top + 1.0)
    .close()
)
hole = hole_prof.revolve(360, (0, 0, 0), (0, 1, 0))

p = W / 2.0 - POST_OFF
for sx in (-1, 1):
    for sy in (-1, 1):
        body = body.union(post.translate((sx * p, sy * p, 0)))
for sx in (-1, 1):
    for sy in (-1, 1):
        body = body.cut(hole.translate((sx * p, sy * p, 0)))

# ---------------- cable hole in the front wall ----------------
side_hole = cq.Solid.makeCylinder(
    SIDE_HOLE_D / 2.0, 4 * T_WALL + 4,
    cq.Vector(0, -W / 2.0 - 2, SIDE_HOLE_Z), cq.Vector(0, 1, 0)
)
body = body.cut(cq.Workplane("XY").add(side_hole))

result = body
